import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # overall width  (X)
H = 132.5          # overall height (Z)
D = 33.5           # overall depth  (Y), open side at -Y, back plate at +Y
T = 1.4            # sheet / wall thickness
R_CORNER = 16.0    # outer radius of the four tube corners (XZ profile)
BACK_A = 4.0       # back edge roll-off length along the depth (Y)
BACK_B = 1.5       # back edge roll-off inset on the back plate
BACK_R_PLATE = 1.2 # blend between roll-off and back plate
BACK_R_WALL = 6.0  # blend between roll-off and side walls

# display window in back plate
WIN_W = 67.8
WIN_H = 36.3
WIN_ZC = 43.0      # window centre height (Z)

# round hole in back plate
HOLE_D = 18.7
HOLE_ZC = -3.4

# relief slot in top wall, at the start of the right-hand corner bend
SLOT_XC = 36.2
SLOT_W = 4.0
SLOT_L = 24.2      # measured from the open front edge to the end of the round

# screw boss on bottom wall, at the front edge
BOSS_R = 3.5
BOSS_L = 8.0
BOSS_ZC = -H / 2 + 2.95
BOSS_HOLE_D = 3.7
BOSS_FILLET = 6.5

# small locating domes on inside of back plate
STUD_D = 2.6
STUD_X = [36.0, 43.5]
STUD_Z = [10.1, -21.0]

# ---------------- body: rounded tube closed at the back ----------------
outer = (
    cq.Workplane("XZ", origin=(0, D / 2, 0))
    .rect(W, H)
    .extrude(D)                      # XZ normal is -Y -> goes from +D/2 to -D/2
    .edges("|Y").fillet(R_CORNER)
)
# back edge: long shallow roll-off (asymmetric chamfer softened by two blends)
outer = outer.faces(">Y").edges().chamfer(BACK_A, BACK_B)
outer = outer.faces(">Y").edges().fillet(BACK_R_PLATE)
outer = outer.edges(
    cq.selectors.BoxSelector((-W, D / 2 - BACK_A - 0.01, -H), (W, D / 2 - BACK_A + 0.01, H))
).fillet(BACK_R_WALL)
body = outer.faces("<Y").shell(-T)

# ---------------- back plate cut-outs ----------------
win = (
    cq.Workplane("XZ", origin=(0, D / 2 + 1, 0))
    .center(0, WIN_ZC)
    .rect(WIN_W, WIN_H)
    .extrude(T + 2)
)
body = body.cut(win)

hole = (
    cq.Workplane("XZ", origin=(0, D / 2 + 1, 0))
    .center(0, HOLE_ZC)
    .circle(HOLE_D / 2)
    .extrude(T + 2)
)
body = body.cut(hole)

# ---------------- relief slot in top wall ----------------
slot_len = SLOT_L + 2.0            # overall slot length incl. round end, starting 2 mm in front
slot = (
    cq.Workplane("XY", origin=(0, 0, H / 2 + 1))
    .center(SLOT_XC, -D / 2 - 2.0 + slot_len / 2)
    .slot2D(slot_len, SLOT_W, angle=90)
    .extrude(-8.0)
)
body = body.cut(slot)

# ---------------- screw boss on bottom wall ----------------
floor_z = -H / 2 + T
y0 = -D / 2
# round-ended cylinder along Y (profile revolved about the boss axis)
boss = (
    cq.Workplane("XY", origin=(0, 0, BOSS_ZC))
    .moveTo(0, y0)
    .lineTo(BOSS_R, y0)
    .lineTo(BOSS_R, y0 + BOSS_L)
    .threePointArc(
        (BOSS_R * 0.7071067811865476, y0 + BOSS_L + BOSS_R * 0.7071067811865476),
        (0, y0 + BOSS_L + BOSS_R),
    )
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
# keep only the part above the outer bottom face (it sits on the floor)
clip = (
    cq.Workplane("XY")
    .box(4 * BOSS_R, BOSS_L + 2 * BOSS_R, 3 * BOSS_R, centered=(True, False, False))
    .translate((0, y0, floor_z - 0.5))
)
boss = boss.intersect(clip)
body = body.union(boss)
# blend the boss into the floor
try:
    body = body.edges(
        cq.selectors.BoxSelector(
            (-BOSS_R - 0.5, y0 + 0.01, floor_z - 0.05),
            (BOSS_R + 0.5, y0 + BOSS_L + BOSS_R + 0.5, floor_z + 0.05),
        )
    ).fillet(BOSS_FILLET)
except Exception:
    pass

boss_hole = (
    cq.Workplane("XZ", origin=(0, y0 - 1, 0))
    .center(0, BOSS_ZC)
    .circle(BOSS_HOLE_D / 2)
    .extrude(-(BOSS_L + 1 - 1.0))
)
body = body.cut(boss_hole)

# ---------------- small locating domes inside back plate ----------------
for sx in STUD_X:
    for sz in STUD_Z:
        dome = (
            cq.Workplane("XY")
            .sphere(STUD_D / 2)
            .translate((sx, D / 2 - T - 0.2, sz))
        )
        body = body.union(dome)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
